import math
import cadquery as cq

# ------------------------------------------------------------------
# Ribbed mounting plate with two front coves and a rear rounded bead.
# Designed lying flat (front/ribbed face up, +z), then stood upright:
#   design x -> world X, design y -> world Z, design z -> world -Y
# ------------------------------------------------------------------

# overall plate
W = 139.2          # width  (world X)
H = 237.3          # height (world Z)
T = 15.2           # thickness (world Y)

# pockets
D = 11.0           # pocket depth from the front face
WALL_SIDE = 2.7    # perimeter wall left/right
WALL_TOP = 2.95    # perimeter wall at top edge

# vertical positions, measured as distance from the top edge
TOP_POCKET = (WALL_TOP, 35.9)
MID_POCKET = (105.3, 157.0)
BOT_POCKET = (162.6, 222.3)

# X-rib cells: (top end, crossing, bottom end) distances from top edge
TOP_X = (0.0, 19.45, 40.0)
MID_X = (102.5, 131.1, 159.7)
BOT_X = (160.2, 192.45, 225.3)

RIB_TOP = 6.0      # diagonal rib widths
RIB_MID = 6.1
RIB_BOT = 6.3
RIB_CENTER = 5.0   # vertical centre rib width

# front coves (cylindrical grooves along X)
COVE1_D, COVE1_R, COVE1_OFF = 55.5, 7.8, 0.0     # upper cove
COVE2_D, COVE2_R, COVE2_OFF = 91.3, 11.3, 1.2    # lower cove (centre inside plate)

# rear bead (rounded rib on the back face)
BEAD_D, BEAD_R, BEAD_CY = 55.5, 19.5, 5.65       # centre depth from front face

# bosses / holes: (x, distance from top, boss radius, hole radius, free-standing)
BOSS_X = 42.0
BOSSES = [
    (-BOSS_X, 30.45, 6.5, 3.6, False),
    (BOSS_X, 30.45, 6.5, 3.6, False),
    (-BOSS_X, 118.1, 8.8, 3.6, False),
    (BOSS_X, 118.1, 8.8, 3.6, False),
    (0.0, 123.0, 10.6, 3.6, False),
    (-41.9, 194.8, 6.6, 3.6, True),
    (41.9, 194.8, 6.6, 3.6, True),
    (0.0, 192.45, 5.6, 3.7, False),   # plain hole at the rib crossing
]
BOSS_ROUND = 0.6   # top rim round on the free-standing bosses


def zc(d):
    """design y coordinate from distance below the top edge"""
    return H / 2.0 - d


def bar(p1, p2, w, h, z0, ext1=0.0, ext2=0.0):
    """rectangular rib between two xy points (extended by ext1 / ext2 at the
    ends), width w, spanning z0 .. z0+h"""
    (x1, y1), (x2, y2) = p1, p2
    L0 = math.hypot(x2 - x1, y2 - y1)
    ux, uy = (x2 - x1) / L0, (y2 - y1) / L0
    L = L0 + ext1 + ext2
    mx = (x1 + x2) / 2.0 + ux * (ext2 - ext1) / 2.0
    my = (y1 + y2) / 2.0 + uy * (ext2 - ext1) / 2.0
    ang = math.degrees(math.atan2(uy, ux))
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .center(mx, my)
        .transformed(rotate=(0, 0, ang))
        .rect(L, w)
        .extrude(h)
    )


# ---------------- base plate ----------------
plate = cq.Workplane("XY").box(W, H, T, centered=(True, True, False)).translate((0, 0, -T))

# rear bead: cylinder along X, keep only the part behind the back face
bead = (
    cq.Workplane("YZ")
    .workplane(offset=-W / 2.0)
    .center(zc(BEAD_D), -BEAD_CY)
    .circle(BEAD_R)
    .extrude(W)
)
bead_clip = cq.Workplane("XY").box(W, 3 * BEAD_R, 2 * BEAD_R, centered=(True, True, False)).translate(
    (0, zc(BEAD_D), -T - 2 * BEAD_R + 0.5)
)
plate = plate.union(bead.intersect(bead_clip))

# front coves
for d, r, off in ((COVE1_D, COVE1_R, COVE1_OFF), (COVE2_D, COVE2_R, COVE2_OFF)):
    cove = (
        cq.Workplane("YZ")
        .workplane(offset=-W / 2.0 - 1)
        .center(zc(d), -off)
        .circle(r)
        .extrude(W + 2)
    )
    plate = plate.cut(cove)

# ---------------- pockets ----------------
xin = W / 2.0 - WALL_SIDE
z0 = -D
hh = D + 1.0


def pocket_region(rng):
    d1, d2 = rng
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .center(0, (zc(d1) + zc(d2)) / 2.0)
        .rect(2 * xin, d2 - d1)
        .extrude(hh)
    )


def x_ribs(cell, w):
    dt, dc, db = cell
    c = (0.0, zc(dc))
    ribs = None
    for sx in (-1, 1):
        for d in (dt, db):
            # from the plate corner of the cell to the crossing point
            b = bar((sx * W / 2.0, zc(d)), c, w, hh + 1, z0 - 0.5, ext1=w, ext2=w / 2.0)
            ribs = b if ribs is None else ribs.union(b)
    return ribs


def center_rib(rng):
    d1, d2 = rng
    return bar((0, zc(d1) + 1), (0, zc(d2) - 1), RIB_CENTER, hh + 1, z0 - 0.5)


def boss_solid(x, d, r, free):
    if free:
        # boss top flush with the front face, small round on its rim
        b = cq.Workplane("XY").workplane(offset=z0 - 0.5).center(x, zc(d)).circle(r).extrude(D + 0.5)
        return b.faces(">Z").edges().fillet(BOSS_ROUND)
    return cq.Workplane("XY").workplane(offset=z0 - 0.5).center(x, zc(d)).circle(r).extrude(hh + 1)


sections = [
    (TOP_POCKET, TOP_X, RIB_TOP, True),
    (MID_POCKET, MID_X, RIB_MID, False),
    (BOT_POCKET, BOT_X, RIB_BOT, True),
]

for rng, cell, w, has_center in sections:
    region = pocket_region(rng)
    keep = x_ribs(cell, w)
    if has_center:
        keep = keep.union(center_rib(rng))
    for (bx, bd, br, hr, free) in BOSSES:
        if rng[0] - br < bd < rng[1] + br:
            keep = keep.union(boss_solid(bx, bd, br, free))
    plate = plate.cut(region.cut(keep))

# ---------------- holes ----------------
for (bx, bd, br, hr, free) in BOSSES:
    th = cq.Workplane("XY").workplane(offset=-T - 1).center(bx, zc(bd)).circle(hr).extrude(T + 2)
    plate = plate.cut(th)

# stand the plate upright: front (ribbed) face toward -Y
result = plate.rotate((0, 0, 0), (1, 0, 0), 90)

VIEW = {"azimuth": 45, "elevation": 26}
